"""Standard hobby servo in a bent bracket.

The servo lies with its long side along X and its output horn facing -Y.  A flat plate is screwed on the
top and on the bottom of the case; from the rear edge of each plate a strap bends 45 degrees away from
the servo and runs back (+Y): the upper strap ends in a round pad with a horn bolt pattern, the lower one
in a split clamp ring with a pinch tab.
"""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# servo case
CORE_W = 40.0        # X length of the servo core (front block)
WING_W = 55.0        # X length over the side wings / ears
BODY_H = 20.4        # Z height of the case
FRONT_D = 9.3        # Y depth of the front block (horn side)
FRONT_R_CHAMFER = (2.1, 4.0)  # steep chamfer of the front-right vertical edge (X, Y)
FRONT_CHAMFER = (4.8, 3.8)   # chamfer of the front-left vertical edge (X, Y)
# small sloped facets at the top / bottom front corners of the front block, each given by three points
# (x, y, depth below the top face) of the cutting plane
CORNER_FACETS = (
    ((-19.4, 3.1, 0.0), (-15.3, 0.0, 0.95), (-9.3, 0.0, 0.0)),
    ((15.8, 0.0, 0.0), (17.9, 0.0, 0.95), (19.9, 3.9, 0.0)),
)
BODY_Y1 = 40.6       # back face of the side wings (Y)
WING_BACK_R = 0.8    # rounding of the wings' rear vertical edges
BACK_RECESS_W = 39.2  # X width of the recess in the back face
BACK_RECESS_D = 4.2   # its depth (Y)
GROOVE_W = 0.6       # seam grooves on the top / bottom faces
GROOVE_D = 0.35

# mounting ears
EAR_Y0 = 6.2         # ear flange front face (Y)
EAR_Y1 = 9.2         # ear flange rear face (Y)
EAR_H = 18.1         # Z height of the ear flange
EAR_R = 1.5
EAR_HOLE_Z = 4.75    # ear holes at +-Z
EAR_HOLE_X = 24.8    # ear holes at +-X
EAR_HOLE_D = 3.0
EAR_CB_D = 4.6
EAR_CB_DEPTH = 1.5
EAR_SLOT_W = 2.3
EAR_GROOVE = (24.0, 1.1, 0.6)  # half-round groove on the ear face between the holes: outer X, radius, depth

# side windows
SMALL_WIN = (10.6, 13.7, 1.8, 7.7)   # near the ears, both sides: Y0, Y1, Z0, Z1
BIG_WIN = (28.9, 34.0, 3.8)          # +X side only: Y0, Y1, half height
BIG_WIN_INNER = (30.0, 31.8, 2.3)    # deeper opening inside it: Y0, Y1, half height
WIN_DEPTH = 1.8

# horn
HORN_X = 10.0
HORN_D = 20.8
HORN_T = 2.4
HORN_Y0 = -8.2       # front face of the horn disc
HUB_D = 8.5
SPLINE_D = 6.2
BOSS_D = 12.0
HORN_HOLE_R = 6.95
HORN_HOLE_D = 2.5
HORN_HOLE_A0 = 20.0  # angle of the first horn hole (deg, from +X towards +Z)
HORN_CENTER_D = 3.0

# bracket plates (top and bottom)
PLATE_W = 55.8
PLATE_Y0 = 21.6
PLATE_Y1 = 41.5
PLATE_T = 4.2
PLATE_R = 5.0
PLATE_HOLE_X = 23.6
PLATE_HOLE_Y = (25.6, 37.6)
PLATE_HOLE_D = 2.8

# arms
ARM_W = 20.0
ARM_T = 3.0
ARM_ZTOP = 27.8      # outer face of the horizontal part of the arm
ARM_Y_START = 39.1   # where the bent part leaves the plate top
ARM_ROOT_R = 3.0     # blend radius between plate top and arm
ARM_HEEL_R = 2.5     # blend radius between plate rear face and arm
END_Y = 76.2         # centre of the arm end / clamp
END_HOLE_D = 7.6
END_SMALL_R = 7.0
END_SMALL_D = 3.0

# clamp on the lower arm
CLAMP_OD = 23.0
CLAMP_ID = 11.0
CLAMP_T = 5.2
CLAMP_DZ = -0.35     # ring centre below the arm mid plane
CLAMP_FLAT = 9.2     # the ring is cut flat this far from its centre (tab side)
CLAMP_TAB_W = 4.8
CLAMP_TAB_Y1 = 89.9
CLAMP_SLOT = 1.0
CLAMP_SCREW_D = 2.4
CLAMP_SCREW_Y = 87.4
RELIEF_D = 2.6
RELIEF_Y = 61.6

H2 = BODY_H / 2.0


def box(x0, x1, y0, y1, z0, z1):
    """axis aligned box between two corners"""
    x0, x1 = min(x0, x1), max(x0, x1)
    y0, y1 = min(y0, y1), max(y0, y1)
    z0, z1 = min(z0, z1), max(z0, z1)
    return cq.Workplane("XY").box(x1 - x0, y1 - y0, z1 - z0).translate(
        ((x0 + x1) / 2, (y0 + y1) / 2, (z0 + z1) / 2)
    )


def cyl_y(x, z, d, y0, y1):
    """cylinder along Y"""
    return cq.Workplane("XZ", origin=(x, max(y0, y1), z)).circle(d / 2).extrude(abs(y1 - y0))


def cyl_z(x, y, d, z0, z1):
    """cylinder along Z"""
    return cq.Workplane("XY", origin=(x, y, min(z0, z1))).circle(d / 2).extrude(abs(z1 - z0))


def cut_all(body, tools):
    """one boolean cut with all the tools at once"""
    return cq.Workplane("XY").add(body.val().cut(*[t.val() for t in tools]))


def fuse_all(body, others):
    """one boolean union of several solids"""
    return cq.Workplane("XY").add(body.val().fuse(*[o.val() for o in others]).clean())


# ---------------- servo case ----------------
front = box(-CORE_W / 2, CORE_W / 2, 0, FRONT_D + 0.5, -H2, H2)


def corner_cut(xc, dx, dy):
    """triangular prism removing the front vertical edge at x = xc (dx points into the block)"""
    return (
        cq.Workplane("XY", origin=(0, 0, -H2 - 1))
        .polyline([(xc - 0.01 * dx / abs(dx), -0.01), (xc + dx, -0.01), (xc - 0.01 * dx / abs(dx), dy)])
        .close()
        .extrude(BODY_H + 2)
    )


front = cut_all(
    front,
    [
        corner_cut(-CORE_W / 2, FRONT_CHAMFER[0], FRONT_CHAMFER[1]),
        corner_cut(CORE_W / 2, -FRONT_R_CHAMFER[0], FRONT_R_CHAMFER[1]),
    ],
)



def facet_cut(pts, zsign):
    """slab outside the plane through three corner points (top face for zsign > 0, bottom for zsign < 0)"""
    p = [cq.Vector(x, y, zsign * (H2 - d)) for x, y, d in pts]
    n = (p[1] - p[0]).cross(p[2] - p[0]).normalized()
    if n.z * zsign < 0:
        n = -n
    xd = (p[2] - p[0]).normalized()
    slab = cq.Workplane(cq.Plane(origin=p[0], xDir=xd, normal=n)).rect(80, 80).extrude(10)
    xs = [v.x for v in p]
    lim = box(min(xs) - 1, max(xs) + 1, -1, 6, zsign * (H2 - 3), zsign * (H2 + 1))
    return cq.Workplane("XY").add(slab.val().intersect(lim.val()))


front = cut_all(front, [facet_cut(f, sz) for f in CORNER_FACETS for sz in (-1, 1)])

wings = box(-WING_W / 2, WING_W / 2, FRONT_D, BODY_Y1, -H2, H2)
wings = wings.edges("|Z and >Y").fillet(WING_BACK_R)

ears = box(-WING_W / 2, WING_W / 2, EAR_Y0, EAR_Y1 + 0.2, -EAR_H / 2, EAR_H / 2)
ears = ears.edges("|Y").fillet(EAR_R)

case = fuse_all(front, [wings, ears])

tools = []
# recess in the back face between the wings
tools.append(box(-BACK_RECESS_W / 2, BACK_RECESS_W / 2, BODY_Y1 - BACK_RECESS_D, BODY_Y1 + 1, -H2 - 1, H2 + 1))
# ear holes: counterbored holes with a slot opening to the outer edge
for sx in (-1, 1):
    for sz in (-1, 1):
        x = sx * EAR_HOLE_X
        z = sz * EAR_HOLE_Z
        tools.append(cyl_y(x, z, EAR_HOLE_D, EAR_Y0 - 0.5, EAR_Y1 + 0.3))
        tools.append(cyl_y(x, z, EAR_CB_D, EAR_Y0 - 1.0, EAR_Y0 + EAR_CB_DEPTH))
        tools.append(box(x, x + sx * 5.0, EAR_Y0 - 1, EAR_Y1 + 0.3, z - EAR_SLOT_W / 2, z + EAR_SLOT_W / 2))
    # shallow half-round groove across the ear face
    tools.append(
        cq.Workplane("YZ", origin=(sx * (CORE_W / 2 + 0.02), EAR_Y0 - EAR_GROOVE[1] + EAR_GROOVE[2], 0))
        .circle(EAR_GROOVE[1])
        .extrude(sx * (EAR_GROOVE[0] - CORE_W / 2 - 0.02))
    )
# shallow windows in the side walls
for sx in (-1, 1):
    xo = sx * WING_W / 2
    for sz in (-1, 1):
        y0, y1, z0, z1 = SMALL_WIN
        tools.append(box(xo - WIN_DEPTH, xo + WIN_DEPTH, y0, y1, sz * z0, sz * z1))
y0, y1, hz = BIG_WIN
tools.append(box(WING_W / 2 - WIN_DEPTH, WING_W / 2 + 1, y0, y1, -hz, hz))
y0, y1, hz = BIG_WIN_INNER
tools.append(box(WING_W / 2 - WIN_DEPTH - 1.5, WING_W / 2 + 1, y0, y1, -hz, hz))
# seam grooves on the top and bottom faces
for sz in (-1, 1):
    zg = sz * H2
    tools.append(box(-CORE_W / 2, CORE_W / 2, FRONT_D - GROOVE_W / 2, FRONT_D + GROOVE_W / 2, zg - GROOVE_D, zg + GROOVE_D))
    for sx in (-1, 1) if sz > 0 else ():
        xg = sx * (BACK_RECESS_W / 2 + GROOVE_W / 2)
        tools.append(box(xg - GROOVE_W / 2, xg + GROOVE_W / 2, FRONT_D, PLATE_Y0 + 1.0, zg - GROOVE_D, zg + GROOVE_D))
case = cut_all(case, tools)

# ---------------- horn ----------------
disc = (
    cq.Workplane("XZ", origin=(HORN_X, HORN_Y0 + HORN_T, 0))
    .circle(HORN_D / 2)
    .extrude(HORN_T)
)
hub = cyl_y(HORN_X, 0, HUB_D, -3.4, HORN_Y0 + HORN_T - 0.1)
spline = cyl_y(HORN_X, 0, SPLINE_D, -0.9, -3.5)
boss = (
    cq.Workplane("XZ", origin=(HORN_X, 0.1, 0))
    .circle(BOSS_D / 2)
    .workplane(offset=1.2)
    .circle(BOSS_D / 2 - 1.6)
    .loft()
)
horn = fuse_all(disc, [hub, spline, boss])
htools = [cyl_y(HORN_X, 0, HORN_CENTER_D, HORN_Y0 - 1, -1.5)]
for i in range(4):
    a = math.radians(HORN_HOLE_A0 + 90 * i)
    htools.append(
        cyl_y(HORN_X + HORN_HOLE_R * math.cos(a), HORN_HOLE_R * math.sin(a), HORN_HOLE_D, HORN_Y0 - 1, HORN_Y0 + HORN_T + 0.5)
    )
horn = cut_all(horn, htools)


# ---------------- plates ----------------
def make_plate(zsign):
    p = box(-PLATE_W / 2, PLATE_W / 2, PLATE_Y0, PLATE_Y1, 0, PLATE_T)
    p = p.edges("|Z").fillet(PLATE_R)
    p = p.faces(">Z").edges().fillet(0.6)
    p = p.faces("<Z").edges().fillet(0.4)
    p = cut_all(p, [cyl_z(sx * PLATE_HOLE_X, y, PLATE_HOLE_D, -1, PLATE_T + 1) for sx in (-1, 1) for y in PLATE_HOLE_Y])
    if zsign > 0:
        return p.translate((0, 0, H2))
    return p.mirror("XY").translate((0, 0, -H2))


# ---------------- arms ----------------
def make_arm():
    """upper strap, built for +Z; the lower strap is its mirror image"""
    ztop = H2 + PLATE_T
    zb = ARM_ZTOP - ARM_T
    off = ARM_T * math.sqrt(2.0)
    y_b = ARM_Y_START + (ARM_ZTOP - ztop)  # end of the upper diagonal line
    y_d = ARM_Y_START + off + (zb - ztop)  # end of the lower diagonal line
    z_in = H2 + 0.8  # the profile is closed inside the plate at this height
    r = ARM_ROOT_R
    t = r * math.tan(math.radians(22.5))
    k = math.sqrt(1.0 + (t / r) ** 2)
    t1 = (ARM_Y_START - t, ztop)
    t2 = (ARM_Y_START + t / math.sqrt(2.0), ztop + t / math.sqrt(2.0))
    mid = (ARM_Y_START - t + t / k, ztop + r - r / k)
    # heel: blend between the plate's rear face (Y = PLATE_Y1) and the inner face of the strap
    zc_heel = ztop + (PLATE_Y1 - ARM_Y_START - off)  # where the inner face meets the rear face
    rh = ARM_HEEL_R
    th = rh * math.tan(math.radians(22.5))
    t3 = (PLATE_Y1, zc_heel - th)
    t4 = (PLATE_Y1 + th / math.sqrt(2.0), zc_heel + th / math.sqrt(2.0))
    eh = rh / math.cos(math.radians(22.5)) - rh
    mid2 = (PLATE_Y1 + eh * 0.9239, zc_heel - eh * 0.3827)
    bent = (
        cq.Workplane("YZ", origin=(-ARM_W / 2, 0, 0))
        .moveTo(t1[0], z_in)
        .lineTo(t1[0], t1[1])
        .threePointArc(mid, t2)
        .lineTo(y_b, ARM_ZTOP)
        .lineTo(y_b + 6.0, ARM_ZTOP)
        .lineTo(y_b + 6.0, zb)
        .lineTo(y_d, zb)
        .lineTo(*t4)
        .threePointArc(mid2, t3)
        .lineTo(PLATE_Y1 - 0.3, z_in)
        .close()
        .extrude(ARM_W)
    )
    flat = (
        cq.Workplane("XY", origin=(0, 0, zb))
        .center(0, (y_b + END_Y) / 2)
        .rect(ARM_W, END_Y - y_b)
        .extrude(ARM_T)
    )
    pad = cyl_z(0, END_Y, ARM_W, zb, ARM_ZTOP)
    return fuse_all(bent, [flat, pad])


top_arm = make_arm()
top_arm = cut_all(
    top_arm,
    [cyl_z(0, END_Y, END_HOLE_D, 0, 40)]
    + [
        cyl_z(dx, END_Y + dy, END_SMALL_D, 0, 40)
        for dx, dy in ((END_SMALL_R, 0), (-END_SMALL_R, 0), (0, END_SMALL_R), (0, -END_SMALL_R))
    ],
)

bot_arm = make_arm().mirror("XY")
zc = -(ARM_ZTOP - ARM_T / 2) + CLAMP_DZ
ring = cut_all(
    cyl_z(0, END_Y, CLAMP_OD, zc - CLAMP_T / 2, zc + CLAMP_T / 2),
    [box(-CLAMP_OD, CLAMP_OD, END_Y + CLAMP_FLAT, END_Y + CLAMP_OD, zc - CLAMP_T, zc + CLAMP_T)],
)
tab = box(-CLAMP_TAB_W / 2, CLAMP_TAB_W / 2, END_Y, CLAMP_TAB_Y1, zc - CLAMP_T / 2, zc + CLAMP_T / 2)
bot_arm = fuse_all(bot_arm, [ring, tab])
bot_arm = cut_all(
    bot_arm,
    [
        cyl_z(0, END_Y, CLAMP_ID, zc - 10, zc + 10),
        box(-CLAMP_SLOT / 2, CLAMP_SLOT / 2, RELIEF_Y, CLAMP_TAB_Y1 + 1, zc - 10, zc + 10),
        cyl_z(0, RELIEF_Y, RELIEF_D, zc - 10, zc + 10),
        cq.Workplane("YZ", origin=(-10, CLAMP_SCREW_Y, zc)).circle(CLAMP_SCREW_D / 2).extrude(20),
    ],
)

result = fuse_all(case, [horn, make_plate(1), make_plate(-1), top_arm, bot_arm])
